import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 175.0          # overall length (X)
W = 100.0          # overall width (Y)
H = 34.0           # overall height (Z)
R_OUT = 5.5        # outer vertical corner radius
R_BOT = 5.0        # outer bottom edge fillet
C_TOP = 0.0        # optional chamfer on the outer rim edge (0 = sharp)

T_RIM = 3.7        # upper wall (rim) thickness
D_UP = 11.9        # depth of upper (thin-wall) section from the rim
T_LOW = 8.3        # lower wall thickness (ledge width = T_LOW - T_RIM)
T_BEV = 6.2        # start of the shallow bevel on the ledge (from outside)
H_BEV = 0.3        # drop of the ledge bevel
R_IN = 5.0         # inner vertical corner radius
T_FLOOR = 4.5      # floor thickness

EMB = 1.2          # toast front-slice relief height (inside floor)
EMB_CRUST = 0.7    # toast crust (side) relief height (inside floor)
EYE_R = 2.1        # eye bump radius (inside)
EYE_H = 0.6        # eye bump height above the toast
EYE_FIL = 0.3      # small round on the eye tops
UND_EMB = 0.7      # underside toast recess depth (front slice)
UND_CRUST = 0.4    # underside toast recess depth (crust)
UND_EYE_R = 3.0    # underside eye dimple radius
UND_EYE_D = 0.5    # underside eye dimple depth (beyond the toast recess)
MOUTH_W = 0.9      # mouth groove width
MOUTH_D = 0.4      # mouth groove depth

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- toast outline (top view, mm, centred on part) -------------
FRONT = [(-17.4, 23.4), (-13.8, 25.5), (-7.8, 24.6), (-1.7, 22.4), (2.1, 20.6),
         (6.7, 23.6), (11.5, 24.6), (16.3, 23.4), (19.3, 21.0), (20.5, 16.8),
         (19.3, 12.6), (18.3, 9.0), (19.9, 2.9), (21.7, -5.5), (22.9, -13.9),
         (23.1, -21.1), (21.5, -24.3), (16.3, -25.0), (-5.3, -25.2),
         (-13.8, -24.8), (-15.6, -22.3), (-16.8, -12.7), (-17.5, -2.0),
         (-17.4, 5.8), (-18.8, 9.2), (-20.4, 13.0), (-20.4, 17.0),
         (-19.4, 20.6)]
CRUST = [(-17.4, 23.4), (-21.0, 22.2), (-23.2, 18.6), (-23.8, 13.8), (-22.8, 8.3),
         (-21.3, 5.3), (-22.2, -3.1), (-23.1, -12.7), (-22.8, -19.9),
         (-20.4, -23.6), (-15.0, -25.0)]
# full silhouette = front slice right/bottom side + crust on the left
FULL = FRONT[:19] + list(reversed(CRUST[1:]))
EYES = [(-5.0, -4.7), (11.1, -4.7)]
MOUTH = ((-4.7, -9.9), (10.3, -9.9))
TONGUE = (-2.0, -11.6)


def rounded_box(lx, ly, h, r, z0=0.0):
    return (cq.Workplane("XY").workplane(offset=z0)
            .rect(lx, ly).extrude(h)
            .edges("|Z").fillet(r))


def spline_prism(pts, h, z0):
    return (cq.Workplane("XY").workplane(offset=z0)
            .spline(pts, periodic=True).close().extrude(h))


def toast_inside(z0):
    """raised toast relief on the inside floor: crust + front slice + eye bumps"""
    t = spline_prism(FULL, EMB_CRUST, z0).union(spline_prism(FRONT, EMB, z0))
    for (x, y) in EYES:
        e = (cq.Workplane("XY").workplane(offset=z0)
             .center(x, y).circle(EYE_R).extrude(EMB + EYE_H))
        e = e.faces(">Z").edges().fillet(EYE_FIL)
        t = t.union(e)
    return t


def toast_underside():
    """shallow toast-shaped recess engraved into the bottom face"""
    t = spline_prism(FULL, UND_CRUST, -0.01).union(
        spline_prism(FRONT, UND_EMB, -0.01))
    for (x, y) in EYES:
        t = t.union(cq.Workplane("XY").center(x, y).circle(UND_EYE_R)
                    .extrude(UND_EMB + UND_EYE_D))
    return t


def face_grooves(z_top, depth):
    """mouth groove + tongue cut downward from z_top"""
    (mx0, my), (mx1, _) = MOUTH
    m = (cq.Workplane("XY").workplane(offset=z_top - depth)
         .center((mx0 + mx1) / 2, my)
         .slot2D(mx1 - mx0, MOUTH_W).extrude(depth + 0.01))
    tg = (cq.Workplane("XY").workplane(offset=z_top - depth)
          .center(TONGUE[0], TONGUE[1])
          .slot2D(3.6, 2.0, angle=90).extrude(depth + 0.01))
    return m.union(tg)


# ---------------- outer body ----------------
body = rounded_box(L, W, H, R_OUT)
body = body.faces("<Z").edges().fillet(R_BOT)

# upper (thin-wall) pocket
up = rounded_box(L - 2 * T_RIM, W - 2 * T_RIM, D_UP + 1.0, R_IN, H - D_UP)
body = body.cut(up)

# lower pocket (thicker walls -> ledge)
low_h = H - D_UP - T_FLOOR
low = rounded_box(L - 2 * T_LOW, W - 2 * T_LOW, low_h + 0.01, R_IN, T_FLOOR)
body = body.cut(low)

# optional small chamfer on the outer top edge of the rim
if C_TOP > 0:
    body = body.faces(">Z").edges(cq.selectors.BoxSelector(
        (-L, -W, H - 0.1), (L, W, H + 0.1))).edges(
        cq.selectors.InverseSelector(cq.selectors.BoxSelector(
            (-(L / 2 - T_RIM) - 0.1, -(W / 2 - T_RIM) - 0.1, H - 0.1),
            ((L / 2 - T_RIM) + 0.1, (W / 2 - T_RIM) + 0.1, H + 0.1)))
    ).chamfer(C_TOP)

# shallow bevel along the inner edge of the ledge (ruled loft, 2 sections)
zl = H - D_UP
s_low = cq.Sketch().rect(L - 2 * T_LOW, W - 2 * T_LOW).vertices().fillet(R_IN)
s_up = (cq.Sketch().rect(L - 2 * T_BEV, W - 2 * T_BEV).vertices().fillet(R_IN)
        .moved(cq.Location(cq.Vector(0, 0, H_BEV + 0.01))))
bev = (cq.Workplane("XY").workplane(offset=zl - H_BEV)
       .placeSketch(s_low, s_up).loft(ruled=True))
body = body.cut(bev)

# ---------------- embossed toast (raised inside, recessed underneath) -------
body = body.union(toast_inside(T_FLOOR - 0.01))
body = body.cut(toast_underside())
body = body.cut(face_grooves(T_FLOOR + EMB, MOUTH_D))
body = body.cut(face_grooves(UND_EMB + MOUTH_D, MOUTH_D))

result = body
